import cadquery as cq

# Switch / connector mounting plate: 4 rectangular switch cut-outs,
# one round connector hole, 4 counterbored U-slots on the X faces and a
# deep pocket on the underside with a cable notch in the +Y face.

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
W = 100.0          # plate size along X
L = 100.0          # plate size along Y
T = 15.0           # plate thickness
R_CORNER = 3.0     # vertical corner radius
F_TOP = 0.5        # top perimeter fillet

# corner U-slots (open to the +/-X faces)
SLOT_DX = 4.9      # slot centre distance from the X faces
SLOT_DY = 11.6     # slot centre distance from the Y faces
SLOT_R = 5.5       # counterbore radius
SLOT_DEPTH = 5.2   # counterbore depth from top
SLOT_HOLE_D = 5.2  # through hole
SLOT_MOUTH_F = 1.5 # rounding where the slot meets the side face

# square (rectangular) switch cut-outs
SQ_W = 18.4        # narrow opening along X
SQ_H = 14.7        # narrow opening along Y
SQ_R = 2.5         # corner radius
SQ_TOP_C = 0.9     # top edge chamfer
SQ_COL_X = -28.4
SQ_PITCH = 30.0
SQ_CB_E = 1.5      # bottom counterbore enlargement per side
SQ_CB_H = 2.5      # bottom counterbore height above recess floor

# central round hole
RH_D = 17.0
RH_SQ = 25.4       # square counterbore from below around round hole
RH_SQ_H = 4.3
RH_SQ_R = 2.0      # corner radius of that counterbore
RH_SQ_DX = -0.4    # small offset of that counterbore from the hole axis
RH_SQ_DY = -0.4

# bottom recess
REC_D = 7.5        # depth of underside recess
RIM_X = 5.5        # rim width along X faces
RIM_YN = 6.5       # rim width along the -Y face
RIM_YP = 4.5       # rim width along the +Y face
REC_R = 2.0        # recess corner radius
BOSS_R = 4.8       # rim bulge radius round the corner holes
DIAG_C = -77.1     # (-X,+Y) corner block: x - y of its 45 deg face
DIAG_X = -39.2     # (-X,+Y) corner block: x of its face parallel to Y

# cable notch in +Y face
NOTCH_X = 0.5
NOTCH_W = 15.0
NOTCH_H = 5.5
NOTCH_F = 1.5      # rounding of the notch's upper corners

# small steps widening the +X rim towards the +Y end
STEP1_Y = 15.0
STEP1_W = 1.0
STEP2_Y = 28.0
STEP2_W = 2.3

# ---------------- base plate ----------------
plate = (
    cq.Workplane("XY")
    .box(W, L, T, centered=(True, True, False))
    .edges("|Z").fillet(R_CORNER)
)

hole_pts = [(sx * (W / 2 - SLOT_DX), sy * (L / 2 - SLOT_DY))
            for sx in (-1, 1) for sy in (-1, 1)]

# ---------------- corner U-slots (straight part + rounded mouth) --------
z0 = T - SLOT_DEPTH
hgt = SLOT_DEPTH + 1
for (px, py) in hole_pts:
    sx = 1 if px > 0 else -1
    edge = sx * W / 2
    ext = (W / 2 - abs(px)) + 2.0
    slot = (
        cq.Workplane("XY", origin=(0, 0, z0))
        .center(px + sx * ext / 2, py).rect(ext, 2 * SLOT_R)
        .extrude(hgt)
    )
    f = SLOT_MOUTH_F
    mouth = (
        cq.Workplane("XY", origin=(0, 0, z0))
        .center(edge + sx * (1.0 - f) / 2, py)
        .rect(f + 1.0, 2 * (SLOT_R + f)).extrude(hgt)
    )
    rounds = (
        cq.Workplane("XY", origin=(0, 0, z0))
        .pushPoints([(edge - sx * f, py + SLOT_R + f),
                     (edge - sx * f, py - SLOT_R - f)])
        .circle(f).extrude(hgt)
    )
    slot = slot.union(mouth.cut(rounds))
    plate = plate.cut(slot)

# top perimeter fillet (also rounds the straight slot walls)
plate = plate.faces(">Z").edges().fillet(F_TOP)

# round end of each slot (sharp edged counterbore) + through hole
for (px, py) in hole_pts:
    plate = plate.cut(
        cq.Workplane("XY", origin=(0, 0, z0))
        .center(px, py).circle(SLOT_R).extrude(hgt)
    )
plate = (
    plate.faces(">Z").workplane()
    .pushPoints([(x, y) for (x, y) in hole_pts])
    .hole(SLOT_HOLE_D)
)

# ---------------- bottom recess ----------------
rec_w = W - 2 * RIM_X
rec_l = L - RIM_YN - RIM_YP
recess = (
    cq.Workplane("XY")
    .center(0, (RIM_YN - RIM_YP) / 2)
    .rect(rec_w, rec_l)
    .extrude(REC_D)
    .edges("|Z").fillet(REC_R)
)
for (y0, dw) in ((STEP1_Y, STEP1_W), (STEP2_Y, STEP2_W)):
    xs = W / 2 - RIM_X - dw
    step = (
        cq.Workplane("XY")
        .center((xs + W / 2 + 1) / 2, (y0 + L / 2 + 1) / 2)
        .rect(W / 2 + 1 - xs, L / 2 + 1 - y0).extrude(REC_D)
    )
    recess = recess.cut(step)
# rim material kept round each corner hole: a disc plus a block
# running from the hole centre out to the plate corner
for (hx, hy) in hole_pts:
    sx = 1 if hx > 0 else -1
    sy = 1 if hy > 0 else -1
    x_in = hx - sx * BOSS_R
    x_out = sx * (W / 2 + 1)
    y_in = hy
    y_out = sy * (L / 2 + 1)
    blk = (
        cq.Workplane("XY")
        .center((x_in + x_out) / 2, (y_in + y_out) / 2)
        .rect(abs(x_out - x_in), abs(y_out - y_in)).extrude(REC_D)
        .union(cq.Workplane("XY").center(hx, hy).circle(BOSS_R)
               .extrude(REC_D))
    )
    recess = recess.cut(blk)

# the (-X,+Y) corner block is cut back along a 45 deg face
diag_blk = (
    cq.Workplane("XY")
    .polyline([(-W / 2 - 1, -W / 2 - 1 - DIAG_C),
               (DIAG_X, DIAG_X - DIAG_C),
               (DIAG_X, L / 2 + 1),
               (-W / 2 - 1, L / 2 + 1)]).close()
    .extrude(REC_D)
)
recess = recess.cut(diag_blk)
plate = plate.cut(recess)

# ---------------- square cut-outs ----------------
sq_pts = [(SQ_COL_X, -SQ_PITCH), (SQ_COL_X, 0.0), (SQ_COL_X, SQ_PITCH),
          (0.0, -SQ_PITCH)]
sq_cut = (
    cq.Workplane("XY").pushPoints(sq_pts)
    .rect(SQ_W, SQ_H).extrude(T + 2).translate((0, 0, -1))
    .edges("|Z").fillet(SQ_R)
)
plate = plate.cut(sq_cut)
for (qx, qy) in sq_pts:
    plate = plate.edges(cq.selectors.BoxSelector(
        (qx - SQ_W / 2 - 0.5, qy - SQ_H / 2 - 0.5, T - 0.2),
        (qx + SQ_W / 2 + 0.5, qy + SQ_H / 2 + 0.5, T + 0.2))).chamfer(SQ_TOP_C)
sq_cb = (
    cq.Workplane("XY").pushPoints(sq_pts)
    .rect(SQ_W + 2 * SQ_CB_E, SQ_H + 2 * SQ_CB_E).extrude(REC_D + SQ_CB_H)
    .edges("|Z").fillet(SQ_R + SQ_CB_E)
)
plate = plate.cut(sq_cb)

# ---------------- round hole ----------------
rh = cq.Workplane("XY").circle(RH_D / 2).extrude(T + 2).translate((0, 0, -1))
plate = plate.cut(rh)
rh_sq = (
    cq.Workplane("XY").center(RH_SQ_DX, RH_SQ_DY)
    .rect(RH_SQ, RH_SQ).extrude(REC_D + RH_SQ_H)
    .edges("|Z").fillet(RH_SQ_R)
)
plate = plate.cut(rh_sq)

# ---------------- cable notch in +Y face ----------------
notch = (
    cq.Workplane("XZ", origin=(0, L / 2 + 1, 0))
    .center(NOTCH_X, (NOTCH_H - 1) / 2)
    .rect(NOTCH_W, NOTCH_H + 1)
    .extrude(RIM_YP + 3)
    .edges("|Y and >Z").fillet(NOTCH_F)
)
plate = plate.cut(notch)

result = plate
